import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 300.0          # plate width  (X)
H = 262.0          # plate height (Z)
T = 8.0            # plate thickness (Y)

WIN_W = 240.0      # window width
WIN_H = 180.0      # window height
WIN_TOP = 30.0     # margin from top edge to window
# (left/right margins are (W-WIN_W)/2, bottom margin is the remainder)

# corner mounting holes (counterbored from the back face)
C_HOLE_D = 7.2
C_CBORE_D = 15.0
C_CBORE_DEPTH = 4.0
C_EDGE_X = 15.0    # from side edges
C_DZ = 105.0       # +/- from window centre (vertical)

# side holes (counterbored from the back face)
S_HOLE_D = 6.6
S_CBORE_D = 11.0
S_CBORE_DEPTH = 6.0
S_EDGE_X = 9.0     # from side edges
S_DZ = 30.0        # +/- from window centre (vertical)

# small plain holes along the bottom edge
SM_HOLE_D = 4.5
SM_EDGE_Z = 7.25                   # from bottom edge
SM_X_FROM_EDGE = [23.5, 41.25, 59.0]  # from each side edge

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
z_top = H / 2.0
z_bot = -H / 2.0
win_cz = z_top - WIN_TOP - WIN_H / 2.0   # window centre height


def back_wp():
    """Workplane on the back face (+Y), normal +Y; local x = X, local y = -Z."""
    return cq.Workplane(
        cq.Plane(origin=(0, T / 2.0, 0), xDir=(1, 0, 0), normal=(0, 1, 0))
    )


def to_back(pts_xz):
    return [(x, -z) for (x, z) in pts_xz]


# ---------------- plate with window ----------------
# plate lies in the XZ plane, thickness along Y, centred on Y = 0
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(T / 2.0, both=True)
)

window = (
    cq.Workplane("XZ")
    .center(0, win_cz)
    .rect(WIN_W, WIN_H)
    .extrude(T, both=True)
)
plate = plate.cut(window)

# ---------------- corner holes (counterbored from back) ----------------
c_pts = to_back([
    (sx * (W / 2.0 - C_EDGE_X), win_cz + sz * C_DZ)
    for sx in (-1, 1) for sz in (-1, 1)
])
plate = plate.cut(
    back_wp().pushPoints(c_pts).circle(C_CBORE_D / 2.0).extrude(-C_CBORE_DEPTH)
)
plate = plate.cut(
    back_wp().pushPoints(c_pts).circle(C_HOLE_D / 2.0).extrude(-T)
)

# ---------------- side holes (counterbored from back) ----------------
s_pts = to_back([
    (sx * (W / 2.0 - S_EDGE_X), win_cz + sz * S_DZ)
    for sx in (-1, 1) for sz in (-1, 1)
])
plate = plate.cut(
    back_wp().pushPoints(s_pts).circle(S_CBORE_D / 2.0).extrude(-S_CBORE_DEPTH)
)
plate = plate.cut(
    back_wp().pushPoints(s_pts).circle(S_HOLE_D / 2.0).extrude(-T)
)

# ---------------- small holes along the bottom ----------------
sm_pts = to_back([
    (sx * (W / 2.0 - d), z_bot + SM_EDGE_Z)
    for d in SM_X_FROM_EDGE for sx in (-1, 1)
])
plate = plate.cut(
    back_wp().pushPoints(sm_pts).circle(SM_HOLE_D / 2.0).extrude(-T)
)

result = plate
